import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# origin: X=0 on the bearing axis, Y=0 on the front face, Z=0 on the underside
DEPTH = 40.6            # overall depth (Y)
BASE_T = 7.2            # base plate thickness
BASE_X0 = -50.6         # base plate left end
BASE_X1 = 34.1          # base plate right end
BASE_R_FL = 5.2         # vertical corner radius, front-left
BASE_R = 4.8            # vertical corner radius, right-hand corners

BLK_X0 = -84.7          # side block (left end)
BLK_X1 = -51.25         # side block (right face)
BLK_Y0 = 26.2           # side block front face
BLK_H = 23.8            # side block height
BLK_FIL = 7.0           # concave fillet block-front / base-end
BLK_HOLE_D = 9.3        # vertical through holes in the side block
BLK_HOLE_DX = 9.55      # half pitch of the block holes
BLK_CONE_R = 5.0        # conical point on the block front face
BLK_CONE_H = 5.0

PIL_R = 21.45           # bearing boss radius (half width)
PIL_ZC = 28.6           # bearing axis height
BORE_R_FRONT = 9.3      # tapered entry radius at the front face
BORE_R_MIN = 4.6        # through-bore (waist) radius
BORE_TAPER_L = 16.0     # length of the front taper
BORE_WAIST_L = 4.0      # length of the waist
BORE_R_BACK = 12.0      # counterbore radius at the back face
BORE_TIP = 118.0        # drill-point angle at the bottom of the back counterbore

SPLIT_X = 4.7           # start of the curved front relief (at the front face)
REC_APEX_X = 19.4       # X where the relief surface is deepest
REC_D = 5.28            # depth of the relief

HOLE_D = 10.5           # base plate through holes
H_FL = (-40.3, 6.9)     # front-left hole
H_BR = (25.1, 33.4)     # back-right hole
H_FR = (7.2, 6.8)       # front-right hole (under the boss)
CB_FR_R = 7.6           # screw-head clearance radius, front-right pocket
CB_BR_R = 7.85          # screw-head clearance radius, back-right channel
CB_FR_TOP = 16.3        # height of the front-right clearance pocket

# ---------------- base plate ----------------
base = (
    cq.Workplane("XY")
    .center((BASE_X0 + BASE_X1) / 2, DEPTH / 2)
    .rect(BASE_X1 - BASE_X0, DEPTH)
    .extrude(BASE_T)
)
base = base.edges("|Z and >X").fillet(BASE_R)
base = base.edges("|Z and <X and <Y").fillet(BASE_R_FL)

# ---------------- side block ----------------
blk = (
    cq.Workplane("XY")
    .center((BLK_X0 + BLK_X1) / 2, (BLK_Y0 + DEPTH) / 2)
    .rect(BLK_X1 - BLK_X0, DEPTH - BLK_Y0)
    .extrude(BLK_H)
)
# bridge between block and base plate with a concave fillet towards the front
bridge = (
    cq.Workplane("XY")
    .moveTo(BLK_X1 - 1.0, DEPTH)
    .lineTo(BLK_X1 - 1.0, BLK_Y0)
    .lineTo(BASE_X0 - BLK_FIL, BLK_Y0)
    .radiusArc((BASE_X0, BLK_Y0 - BLK_FIL), BLK_FIL)
    .lineTo(BASE_X0 + 1.0, BLK_Y0 - BLK_FIL)
    .lineTo(BASE_X0 + 1.0, DEPTH)
    .close()
    .extrude(BASE_T)
)

# ---------------- bearing boss ----------------
pil = (
    cq.Workplane("XZ")
    .moveTo(-PIL_R, BASE_T)
    .lineTo(PIL_R, BASE_T)
    .lineTo(PIL_R, PIL_ZC)
    .threePointArc((0, PIL_ZC + PIL_R), (-PIL_R, PIL_ZC))
    .close()
    .extrude(-DEPTH)
)

body = base.union(blk).union(bridge).union(pil)

# curved relief on the right half of the boss front (vertical cylindrical surface)
rc = ((REC_APEX_X - SPLIT_X) ** 2 + REC_D ** 2) / (2 * REC_D)
rel = (
    cq.Workplane("XY")
    .workplane(offset=BASE_T)
    .center(REC_APEX_X, REC_D - rc)
    .circle(rc)
    .extrude(PIL_ZC + PIL_R)
)
rel_box = (
    cq.Workplane("XY")
    .workplane(offset=BASE_T)
    .center((SPLIT_X + PIL_R + 5) / 2, 0)
    .rect(PIL_R + 5 - SPLIT_X, 2 * REC_D + 0.01)
    .extrude(PIL_ZC + PIL_R)
)
body = body.cut(rel.intersect(rel_box))

# bore: long tapered entry, short waist, back counterbore with drill point
y1 = BORE_TAPER_L
y2 = y1 + BORE_WAIST_L
y3 = y2 + (BORE_R_BACK - BORE_R_MIN) / math.tan(math.radians(BORE_TIP / 2))
bore = (
    cq.Workplane("XY")
    .moveTo(0, -1)
    .lineTo(BORE_R_FRONT, -1)
    .lineTo(BORE_R_FRONT, 0)
    .lineTo(BORE_R_MIN, y1)
    .lineTo(BORE_R_MIN, y2)
    .lineTo(BORE_R_BACK, y3)
    .lineTo(BORE_R_BACK, DEPTH + 1)
    .lineTo(0, DEPTH + 1)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((0, 0, PIL_ZC))
)
body = body.cut(bore)

# base plate through holes
for (hx, hy) in (H_FL, H_BR, H_FR):
    body = body.cut(
        cq.Workplane("XY").workplane(offset=-1).center(hx, hy).circle(HOLE_D / 2).extrude(BASE_T + 2)
    )

# screw-head clearance: low pocket at the front-right, full-height channel at the back-right
body = body.cut(
    cq.Workplane("XY").workplane(offset=BASE_T).center(*H_FR).circle(CB_FR_R).extrude(CB_FR_TOP - BASE_T)
)
body = body.cut(
    cq.Workplane("XY").workplane(offset=BASE_T).center(*H_BR).circle(CB_BR_R).extrude(PIL_ZC + PIL_R)
)

# side block holes
bx = (BLK_X0 + BLK_X1) / 2
by = (BLK_Y0 + DEPTH) / 2
for dx in (-BLK_HOLE_DX, BLK_HOLE_DX):
    body = body.cut(
        cq.Workplane("XY").workplane(offset=-1).center(bx + dx, by).circle(BLK_HOLE_D / 2).extrude(BLK_H + 2)
    )

# conical point protruding from the side block front face
cone = cq.Solid.makeCone(
    BLK_CONE_R, 0.0, BLK_CONE_H,
    pnt=cq.Vector(bx, BLK_Y0, BLK_H / 2),
    dir=cq.Vector(0, -1, 0),
)
body = body.union(cq.Workplane("XY").add(cone))

result = body
